import math
import cadquery as cq

# ---------------------------------------------------------------
# Light freighter ("saucer with twin mandibles")
# X = beam (cockpit on -X side), Y = length (mandibles point -Y), Z = up
# origin at the centre of the round hull, mid height
# ---------------------------------------------------------------

# ---- main disc ----
R = 73.7          # disc radius
RIM_H = 5.6       # half height of the vertical rim
BEVEL_W = 12.0    # radial width of the rim bevel
SHOULDER_H = 10.8 # half height just inside the bevel
DOME_H = 12.0     # half height at the centre

# ---- front hull (between disc and mandibles) ----
FRONT_Y = -84.0   # front face of the hull between the mandibles
FRONT_H = 5.0     # half height of the hull where it meets the mandibles
FRONT_TOP_H = 11.6
FRONT_INSET = 12.0

# ---- mandibles ----
TIP_Y = -126.3
SLOT_HW = 11.2    # half width of the slot between the mandibles
TIP_OUT = 24.0    # outer x of a mandible tip
MAND_H = 4.7      # half thickness of a mandible
MAND_EDGE_H = 2.2 # half thickness at the outer edge of the mandible wing
MAND_Y1 = -78.0   # where the mandibles run into the hull
MAND_OUT_X = 49.5 # outer x of the mandible wing at its root

# ---- docking band across the beam ----
DOCK_YC = -1.6
DOCK_HW = 12.6    # half width (Y)
DOCK_H = 16.0     # half height
DOCK_CH_Y = 4.5   # chamfers of the octagonal section
DOCK_CH_Z = 4.0
DOCK_X = 59.0     # half length of the full-size part
DOCK_END_X = 70.2 # half length of the band
DOCK_END_R = 10.4 # the band ends blend into this circle
PORT_R = 9.7      # docking port radius
PORT_X = 71.0     # outer face of the port

# ---- central spine ----
SPINE_X0 = -19.0  # starboard edge of the spine
SPINE_X1 = 9.7    # port edge of the spine
SPINE_RIDGE_X = 1.0
SPINE_XC = (SPINE_X0 + SPINE_X1) / 2
SPINE_HW = (SPINE_X1 - SPINE_X0) / 2
SPINE_REAR_Y = 66.0
SPINE_KEEL_F = 1.04   # underside of the spine is slightly deeper

# ---- keel bump under the forward spine ----
KEEL_Y0 = -63.0
KEEL_Y1 = -37.0
KEEL_H = 17.2

# ---- cockpit tube (starboard = -X) ----
CP_X = -68.6
CP_Z = 2.5
CP_R = 8.5        # cockpit tube radius
CP_Y0 = -12.0
CP_Y1 = -54.0     # start of the conical nose
CP_TIP_Y = -67.8
CP_TIP_R = 4.6
CP_NECK_X = -55.5 # inner end of the neck joining the tube to the hull
CP_NECK_Y1 = -50.0

# ---- radar dish (port side, top) ----
DISH_X = 33.5
DISH_Y = -37.0
DISH_Z = 25.3
DISH_R = 9.9
DISH_APEX = 34.6
PED_BASE_HW = 13.0  # half width of the dish pedestal at the hull
PED_TOP_HW = 4.5

# ---- raised blocks along the stern rim ----
STERN_Y0 = 48.0
STERN_LOW_H = 10.0
STERN_PEAK_H = 13.0
STERN_EAVE_H = 5.5
STERN_BLOCKS = [(-28.0, 9.0, 62.0), (-11.0, 9.0, 67.5), (11.0, 10.0, 67.5)]  # (x, half width, y of peak)

# ---- turrets ----
TUR_X = 12.4
TUR_Y = 23.8
TUR_R = 5.8


def ruled_slab(pts, h_side, h_top, inset):
    """Polygon slab: vertical sides +-h_side, bevelled to +-h_top."""
    w_full = cq.Wire.makePolygon([cq.Vector(x, y, 0) for x, y in pts], close=True)
    w_in = w_full.offset2D(-inset, "intersection")[0]
    secs = [
        w_in.translate(cq.Vector(0, 0, -h_top)),
        w_full.translate(cq.Vector(0, 0, -h_side)),
        w_full.translate(cq.Vector(0, 0, h_side)),
        w_in.translate(cq.Vector(0, 0, h_top)),
    ]
    return cq.Workplane("XY").add(cq.Solid.makeLoft(secs, True))


def side_profile(prof, x0=-90.0, x1=90.0):
    """Extrude a (y, z) profile along X between x0 and x1."""
    return (
        cq.Workplane("YZ", origin=(x0, 0, 0))
        .polyline(prof).close()
        .extrude(x1 - x0)
    )


def mirror_z(pts):
    """(y, z) upper half profile (front to back) -> closed symmetric profile."""
    return [(y, -z) for y, z in pts] + [(y, z) for y, z in pts[::-1]]


# ---------------- main disc ----------------
disc = (
    cq.Workplane("XZ")
    .polyline([
        (0, -DOME_H),
        (R - BEVEL_W, -SHOULDER_H),
        (R, -RIM_H),
        (R, RIM_H),
        (R - BEVEL_W, SHOULDER_H),
        (0, DOME_H),
    ])
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
# the forward part of the round hull is replaced by the front hull
disc = disc.intersect(
    cq.Workplane("XY").box(3 * R, 2 * R, 4 * DOME_H)
    .translate((0, DOCK_YC - DOCK_HW + 1.0 + R, 0))
)
# notches where the docking band ends sit
for sx in (-1, 1):
    disc = disc.cut(
        cq.Workplane("XY")
        .box(10, 2 * DOCK_HW - 1.0, 4 * DOME_H)
        .translate((sx * (DOCK_END_X + 4.7), DOCK_YC, 0))
    )

# ---------------- front hull ----------------
front_half = [(47.7, FRONT_Y), (56.1, -65.2), (60.5, -47.0), (67.7, -39.8),
              (69.8, -28.2), (70.9, DOCK_YC - 2.0)]
front_pts = [(-x, y) for x, y in front_half[::-1]] + front_half
front_slab = ruled_slab(front_pts, RIM_H, FRONT_TOP_H, FRONT_INSET)
front_prof = mirror_z([(FRONT_Y - 1, FRONT_H), (-74, 9.6), (-58, 10.8), (-45, 11.2),
                       (-28, FRONT_TOP_H), (0, FRONT_TOP_H)])
front = front_slab.intersect(side_profile(front_prof))

# ---------------- mandibles ----------------
def mandible(sign):
    # inner bar with a squared-off tip
    bar = (
        cq.Workplane("XY")
        .box(TIP_OUT - SLOT_HW, MAND_Y1 - TIP_Y, 2 * MAND_H)
        .translate((sign * (TIP_OUT + SLOT_HW) / 2, (MAND_Y1 + TIP_Y) / 2, 0))
        .edges("|Y").chamfer(0.8)
    )
    # outer wing: triangular in plan, thinning towards its outer edge
    plan = (
        cq.Workplane("XY", origin=(0, 0, -MAND_H))
        .polyline([(sign * (TIP_OUT - 0.5), TIP_Y), (sign * MAND_OUT_X, MAND_Y1),
                   (sign * (TIP_OUT - 0.5), MAND_Y1)]).close()
        .extrude(2 * MAND_H)
    )
    sect = (
        cq.Workplane("XZ", origin=(0, MAND_Y1 + 1, 0))
        .polyline([(sign * TIP_OUT, -MAND_H), (sign * (MAND_OUT_X + 1), -MAND_EDGE_H),
                   (sign * (MAND_OUT_X + 1), MAND_EDGE_H), (sign * TIP_OUT, MAND_H)]).close()
        .extrude(MAND_Y1 + 2 - TIP_Y)
    )
    return bar.union(plan.intersect(sect))

mand = mandible(1).union(mandible(-1))

# ---------------- docking band ----------------
cy, cz = DOCK_CH_Y, DOCK_CH_Z
dock_sec = [
    (-DOCK_HW + cy, -DOCK_H), (DOCK_HW - cy, -DOCK_H), (DOCK_HW, -DOCK_H + cz),
    (DOCK_HW, DOCK_H - cz), (DOCK_HW - cy, DOCK_H), (-DOCK_HW + cy, DOCK_H),
    (-DOCK_HW, DOCK_H - cz), (-DOCK_HW, -DOCK_H + cz),
]
dock = (
    cq.Workplane("YZ", origin=(-DOCK_X, 0, 0))
    .polyline([(DOCK_YC + y, z) for y, z in dock_sec]).close()
    .extrude(2 * DOCK_X)
)


def dock_end(sign):
    """Band end: octagon blending into the round docking port."""
    oct_w = cq.Wire.makePolygon(
        [cq.Vector(sign * DOCK_X, DOCK_YC + y, z) for y, z in dock_sec], close=True)
    circ = cq.Wire.makeCircle(DOCK_END_R, cq.Vector(sign * DOCK_END_X, DOCK_YC, 0),
                              cq.Vector(sign, 0, 0))
    taper = cq.Solid.makeLoft([oct_w, circ], True)
    port = cq.Solid.makeCylinder(PORT_R, PORT_X - DOCK_END_X + 0.5,
                                 cq.Vector(sign * (DOCK_END_X - 0.5), DOCK_YC, 0),
                                 cq.Vector(sign, 0, 0))
    return cq.Workplane("XY").add(taper).union(cq.Workplane("XY").add(port))

dock = dock.union(dock_end(1)).union(dock_end(-1))

# ---------------- central spine ----------------
# gabled ridge running fore and aft; (y, ridge height, eave height) stations
SPINE_STATIONS = [
    (FRONT_Y, 8.5, 6.0),
    (-47.0, 13.7, 10.5),
    (-28.0, 16.3, 12.2),
    (-4.0, 20.0, 15.5),
    (10.0, 15.5, 14.0),
    (59.0, 13.8, 12.9),
    (SPINE_REAR_Y, 13.3, 12.4),
]


def spine_section(y, ridge, eave, deep):
    k = SPINE_KEEL_F if deep else 1.0
    pts = [(SPINE_X0, -eave * k), (SPINE_RIDGE_X, -ridge * k), (SPINE_X1, -eave * k),
           (SPINE_X1, eave), (SPINE_RIDGE_X, ridge), (SPINE_X0, eave)]
    return cq.Wire.makePolygon([cq.Vector(x, y, z) for x, z in pts], close=True)


spine = cq.Workplane("XY").add(cq.Solid.makeLoft(
    [spine_section(y, p, e, True) for y, p, e in SPINE_STATIONS], True))

# keel bump under the forward spine
keel = (
    cq.Workplane("XY")
    .box(2 * SPINE_HW - 8, KEEL_Y1 - KEEL_Y0, KEEL_H)
    .translate((SPINE_XC, (KEEL_Y0 + KEEL_Y1) / 2, -KEEL_H / 2))
    .edges("|X and <Z").chamfer(3.0)
)

# gabled ramp blocks along the stern rim (top side)
def stern_block(xc, hw, y_peak):
    roof = (
        cq.Workplane("XZ", origin=(0, R + 1.0, 0))
        .polyline([(xc - hw, 0.0), (xc - hw, STERN_EAVE_H), (xc, STERN_PEAK_H + 1.0),
                   (xc + hw, STERN_EAVE_H), (xc + hw, 0.0)]).close()
        .extrude(R + 1.0 - STERN_Y0)
    )
    ramp = side_profile([(STERN_Y0, 0.0), (STERN_Y0, STERN_LOW_H), (y_peak, STERN_PEAK_H),
                         (R + 1.0, STERN_PEAK_H - 4.0), (R + 1.0, 0.0)], xc - hw - 1, xc + hw + 1)
    rim = cq.Workplane("XY").circle(R - 0.4).extrude(STERN_PEAK_H + 2)
    return roof.intersect(ramp).intersect(rim)

fins = None
for xc, hw, yp in STERN_BLOCKS:
    b = stern_block(xc, hw, yp)
    fins = b if fins is None else fins.union(b)

# ---------------- cockpit ----------------
cp_prof = [
    (0, CP_Y0), (CP_R, CP_Y0), (CP_R, CP_Y1), (CP_TIP_R, CP_TIP_Y), (0, CP_TIP_Y),
]
cockpit = (
    cq.Workplane("XY")
    .polyline(cp_prof).close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .translate((CP_X, 0, CP_Z))
)
cockpit = cockpit.faces("<Y").edges().fillet(2.5)
neck = (
    cq.Workplane("XY")
    .box(CP_NECK_X - CP_X, CP_Y0 - 0.6 - CP_NECK_Y1, 2 * CP_R - 0.4)
    .translate(((CP_X + CP_NECK_X) / 2, (CP_Y0 - 0.6 + CP_NECK_Y1) / 2, CP_Z))
)

# ---------------- radar dish ----------------
dish_disk = (
    cq.Workplane("XZ", origin=(DISH_X, DISH_Y + 15, DISH_Z))
    .circle(DISH_R).extrude(30)
)
# side profile of the dish: the face leans forwards, the back is nearly upright
dish_wedge = side_profile(
    [(DISH_Y - 13.2, 6.0), (DISH_Y + 10.0, 6.0), (DISH_Y + 9.6, 9.9), (DISH_Y + 8.0, 20.3),
     (DISH_Y + 4.0, DISH_APEX), (DISH_Y + 3.4, DISH_APEX)],
    DISH_X - 20, DISH_X + 20)
dish = dish_disk.intersect(dish_wedge)
# tapered pedestal under the dish (same side profile as the dish wedge)
ped_front = (
    cq.Workplane("XZ", origin=(0, DISH_Y + 20, 0))
    .polyline([(DISH_X - PED_BASE_HW, 6.0), (DISH_X + PED_BASE_HW, 6.0),
               (DISH_X + PED_TOP_HW, DISH_Z - 6.0), (DISH_X - PED_TOP_HW, DISH_Z - 6.0)]).close()
    .extrude(40)
)
ped_side = side_profile(
    [(DISH_Y - 9.0, 6.0), (DISH_Y + 10.0, 6.0), (DISH_Y + 8.5, DISH_Z - 6.0),
     (DISH_Y + 1.0, DISH_Z - 6.0)],
    DISH_X - 20, DISH_X + 20)
dish = dish.union(ped_front.intersect(ped_side))

# ---------------- turrets ----------------
turrets = (
    cq.Workplane("XY", origin=(TUR_X, TUR_Y, -DOME_H - 2.0)).circle(TUR_R)
    .extrude(2 * DOME_H + 4.0)
    .edges().chamfer(1.0)
)

result = (
    disc.union(front).union(mand).union(dock)
    .union(spine).union(keel).union(fins)
    .union(cockpit).union(neck).union(dish).union(turrets)
)

VIEW = {"azimuth": 45, "elevation": 26}
